import math

import cadquery as cq

# ---------------------------------------------------------------------------
# Pair of domed knob caps with a hex socket through the crown and a keyed
# double-D bore in a central boss underneath.  All sizes in millimetres.
# ---------------------------------------------------------------------------
R = 20.0            # outer dome radius
Z0 = -0.15          # dome centre sits a hair below the base plane
PITCH = 51.0        # centre distance of the two caps (along Y)

HEX_AF = 9.5        # hex socket across flats (through the crown)

SHELL_R = 18.5      # inner (spherical) radius of the dome wall
BOSS_R = 15.4       # outer radius of the central boss
BORE_R = 14.4       # bore radius
FLAT_X = 10.18      # half distance across the two bore flats
BORE_D = 10.9       # depth of the keyed bore
CHAMBER_R = 15.0    # slightly wider chamber above the bore (between the flats)
CHAMBER_D = 12.1    # chamber ceiling height
POCKET_D = 13.2     # deeper ceiling over the -Y part of the chamber
POCKET_Y = 1.8      # y position of that ceiling step
CB_R = 14.9         # shallow counterbore at the bore mouth
CB_D = 0.4

RIM_STEP_R = 19.3   # small relief step on the underside rim
RIM_STEP_D = 0.02

NOTCH_W = 3.6       # key notch in the bore mouth (at +Y)
NOTCH_H = 2.8

SLIT_R = 15.5       # radius of the hairline slit that breaks through the dome
SLIT_W = 0.03       # slit width
SLIT_Z0 = 8.0
SLIT_A0 = 50.0      # slit start angle (deg, from +X)
SLIT_A1 = 229.0     # slit end angle

VIEW = {"azimuth": 45, "elevation": 26}


def sphere_solid(r, zc):
    """Sphere whose poles and seam lie below the base plane (clean dome face)."""
    s = cq.Solid.makeSphere(r, angleDegrees1=-90, angleDegrees2=90)
    return (
        cq.Workplane("XY")
        .add(s)
        .rotate((0, 0, 0), (0, 1, 0), 90)
        .rotate((0, 0, 0), (0, 0, 1), 45)
        .translate((0, 0, zc))
    )


def upper_half(wp):
    return wp.intersect(cq.Workplane("XY").box(3 * R, 3 * R, 2 * R, centered=(True, True, False)))


def double_d(wp, r, fx):
    """Closed double-D outline: arcs on +/-Y, flats at x = +/-fx."""
    h = math.sqrt(r * r - fx * fx)
    return (
        wp.moveTo(fx, -h)
        .lineTo(fx, h)
        .threePointArc((0, r), (-fx, h))
        .lineTo(-fx, -h)
        .threePointArc((0, -r), (fx, -h))
        .close()
    )


def sector_prism(a0, a1, z0, height, rad=40.0):
    """Wedge covering the polar sector a0..a1 (degrees)."""
    pts = [(0, 0)]
    n = 4
    for i in range(n + 1):
        a = math.radians(a0 + (a1 - a0) * i / n)
        pts.append((rad * math.cos(a), rad * math.sin(a)))
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(height)


def make_cap():
    # solid hemispherical dome
    cap = upper_half(sphere_solid(R, Z0))

    # hollow it: spherical recess between the dome wall and the central boss
    inner = upper_half(sphere_solid(SHELL_R, Z0))
    boss = cq.Workplane("XY").circle(BOSS_R).extrude(2 * R).rotate((0, 0, 0), (0, 0, 1), 135)
    cap = cap.cut(inner.cut(boss))

    # shallow relief step on the underside rim
    cap = cap.cut(cq.Workplane("XY").circle(RIM_STEP_R).circle(SHELL_R - 0.5).extrude(RIM_STEP_D))

    # double-D keyed bore in the boss
    cap = cap.cut(double_d(cq.Workplane("XY"), BORE_R, FLAT_X).extrude(BORE_D))

    # slightly wider chamber above the bore, still bounded by the flats
    chamber = (
        cq.Workplane("XY")
        .workplane(offset=BORE_D - 0.01)
        .circle(CHAMBER_R)
        .extrude(CHAMBER_D - BORE_D + 0.01)
        .rotate((0, 0, 0), (0, 0, 1), 135)
        .intersect(cq.Workplane("XY").box(2 * FLAT_X, 3 * R, 3 * R))
    )
    cap = cap.cut(chamber)

    # deeper ceiling over the -Y part of the chamber
    deep = (
        double_d(cq.Workplane("XY"), BORE_R, FLAT_X)
        .extrude(POCKET_D)
        .intersect(cq.Workplane("XY").center(0, POCKET_Y - 20).box(3 * R, 40, 3 * R))
    )
    cap = cap.cut(deep)

    # shallow round counterbore at the bore mouth
    cap = cap.cut(cq.Workplane("XY").circle(CB_R).extrude(CB_D).rotate((0, 0, 0), (0, 0, 1), 135))

    # key notch through the boss wall at +Y
    notch = cq.Workplane("XY").center(0, BORE_R + 0.5).box(NOTCH_W, 3.0, NOTCH_H, centered=(True, True, False))
    cap = cap.cut(notch)

    # hex socket through the crown (corners on +/-Y)
    hexcut = (
        cq.Workplane("XY")
        .polygon(6, HEX_AF / math.cos(math.pi / 6))
        .extrude(2 * R)
        .rotate((0, 0, 0), (0, 0, 1), 30)
    )
    cap = cap.cut(hexcut)

    # hairline flex slit around half of the boss, breaking out through the dome
    slit = (
        cq.Workplane("XY")
        .workplane(offset=SLIT_Z0)
        .circle(SLIT_R + SLIT_W)
        .circle(SLIT_R)
        .extrude(6.0)
        .intersect(sector_prism(SLIT_A0, SLIT_A1, SLIT_Z0, 6.0))
    )
    cap = cap.cut(slit)
    return cap


cap = make_cap()
result = cap.translate((0, -PITCH / 2, 0)).union(cap.translate((0, PITCH / 2, 0)))
